"""Flanged cylindrical cup / bell-mouth bushing.

Axis along X.  Rear face (x = -L/2): thin outer wall, deep annular recess and a
central boss carrying the through hole.  Front face (x = +L/2): flange whose
face is a smooth S-shaped bell-mouth (trumpet) dish leading into a bore that
ends on a flat floor with the through hole.  Concave fillet between the body
and the back of the flange.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 75.5            # overall length along X
R_BODY = 50.0       # body outer radius
R_FL = 55.15        # flange outer radius
T_FL = 4.9          # flange thickness
FIL_FL = 4.8        # concave fillet between body and flange

# front bell-mouth dish (S-shaped profile, tangent to the flange face)
R_BORE = 15.7       # bore radius (where the dish ends)
DISH_D = 20.0       # depth of the dish at the bore edge
R_INF = 22.0        # radius of the inflection (steepest point) of the dish
PHI_M = 55.0        # steepest slope of the dish (deg from the face plane)
PHI_E = 45.0        # slope of the dish where it meets the bore (deg)
BORE_D = 36.5       # depth of the bore floor from the front face
R_HOLE = 7.9        # through hole radius

# rear recess / boss
R_BOSS = 27.5       # boss radius
R_REC = 45.2        # recess outer radius (outer wall inner radius)
REC_D = 58.0        # recess depth from the rear face

x0 = -L / 2.0       # rear face
x1 = L / 2.0        # front face

V = cq.Vector


def seg(a, b):
    return cq.Edge.makeLine(V(a[0], a[1], 0), V(b[0], b[1], 0))


# ---------------- dish profile ----------------
# Analytic S-curve: flat ring -> convex arc (radius RHO1, tangent to the face)
# -> inflection at R_INF with slope PHI_M -> concave arc (radius R2) -> bore
# edge at depth DISH_D with slope PHI_E.  It is realised as one smooth spline
# interpolating the analytic curve (positions and tangents) at a few stations.
_pm, _pe = math.radians(PHI_M), math.radians(PHI_E)
R2 = (R_INF - R_BORE) / (math.sin(_pm) - math.sin(_pe))
DX2 = R2 * (math.cos(_pe) - math.cos(_pm))
RHO1 = (DISH_D - DX2) / (1.0 - math.cos(_pm))
R_T = R_INF + RHO1 * math.sin(_pm)          # where the dish leaves the face
D_INF = RHO1 * (1.0 - math.cos(_pm))


def dish_depth_slope(r):
    """depth below the front face and slope (rad) of the dish at radius r"""
    if r >= R_T:
        return 0.0, 0.0
    if r >= R_INF:
        ph = math.asin((R_T - r) / RHO1)
        return RHO1 * (1.0 - math.cos(ph)), ph
    ph = math.asin(math.sin(_pm) - (R_INF - r) / R2)
    return D_INF + R2 * (math.cos(ph) - math.cos(_pm)), ph


stations = [R_FL, R_T, 0.5 * (R_T + R_INF) + 4.0, 0.5 * (R_T + R_INF) - 4.0,
            R_INF, R_BORE]
sp_pts, sp_tan = [], []
for r in stations:
    d, ph = dish_depth_slope(r)
    sp_pts.append(V(x1 - d, r, 0))
    sp_tan.append(V(-math.sin(ph), -math.cos(ph), 0))
dish = cq.Edge.makeSpline(sp_pts, tangents=sp_tan, scale=True)

# ---------------- half cross-section (X axial, Y radial) ----------------
outer = [
    (x0, R_HOLE),
    (x0, R_BOSS),
    (x0 + REC_D, R_BOSS),
    (x0 + REC_D, R_REC),
    (x0, R_REC),
    (x0, R_BODY),
    (x1 - T_FL, R_BODY),
    (x1 - T_FL, R_FL),
    (x1, R_FL),
]
inner = [
    (x1 - DISH_D, R_BORE),
    (x1 - BORE_D, R_BORE),
    (x1 - BORE_D, R_HOLE),
    (x0, R_HOLE),
]
edges = [seg(outer[i], outer[i + 1]) for i in range(len(outer) - 1)]
edges.append(dish)
edges += [seg(inner[i], inner[i + 1]) for i in range(len(inner) - 1)]

profile = cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))
solid = cq.Solid.revolve(profile, 360, V(0, 0, 0), V(1, 0, 0))

# concave fillet where the body meets the back of the flange
fl_edges = [
    e for e in solid.Edges()
    if e.geomType() == "CIRCLE"
    and abs(e.Center().x - (x1 - T_FL)) < 1e-3
    and abs(e.radius() - R_BODY) < 1e-3
]
solid = solid.fillet(FIL_FL, fl_edges)

result = cq.Workplane("XY").add(solid)
